import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 171.6          # plate width  (X)
H = 237.0          # plate height (Z)
T = 4.7            # plate thickness (Y)
R_LEFT = 19.5      # corner radius, left (-X) side
R_RIGHT = 29.0     # corner radius, right (+X) side
FRONT_ROUND = 0.8  # round on the front perimeter edge
BACK_ROUND = 0.3   # round on the back perimeter edge

GROOVE_INSET = 6.4   # top/bottom distance from plate edge to outer edge of the C-groove
GROOVE_INSET_R = 7.2 # right-side distance from plate edge to outer edge of the C-groove
GROOVE_W = 16.2      # width of the top/bottom legs of the C-groove
GROOVE_W_R = 16.1    # width of the right-hand leg of the C-groove
GROOVE_XL = 17.0     # distance from plate left edge to the closed end of the groove
GROOVE_R_OUT = 22.0  # outer corner radius of the groove
GROOVE_R_IN = 12.5   # inner corner radius of the groove
GROOVE_END_R = 1.8   # small radius on the groove end corners
GROOVE_D = 1.5       # groove depth into the front face

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate ----------------
# plate lies in the XZ plane, front face at y = 0, back face at y = +T
plate = (
    cq.Workplane("XZ")
    .rect(W, H)
    .extrude(-T)          # XZ normal is -Y, so negative extrude goes to +Y
)
plate = plate.edges("|Y and <X").fillet(R_LEFT)
plate = plate.edges("|Y and >X").fillet(R_RIGHT)
plate = plate.faces("<Y").edges().fillet(FRONT_ROUND)
plate = plate.faces(">Y").edges().fillet(BACK_ROUND)

# ---------------- C-shaped groove cut into the front face ----------------
x_left = -W / 2 + GROOVE_XL
x_right = W / 2 - GROOVE_INSET_R
z_top = H / 2 - GROOVE_INSET

outer = (
    cq.Workplane("XZ", origin=(0, -1.0, 0))
    .center((x_left + x_right) / 2, 0)
    .rect(x_right - x_left, 2 * z_top)
    .extrude(-(GROOVE_D + 1.0))      # from y=-1 to y=GROOVE_D
)
outer = outer.edges("|Y and >X").fillet(GROOVE_R_OUT)
outer = outer.edges("|Y and <X").fillet(GROOVE_END_R)

in_right = x_right - GROOVE_W_R
in_top = z_top - GROOVE_W
in_left = x_left - 5.0
inner = (
    cq.Workplane("XZ", origin=(0, -2.0, 0))
    .center((in_left + in_right) / 2, 0)
    .rect(in_right - in_left, 2 * in_top)
    .extrude(-(GROOVE_D + 3.0))
)
inner = inner.edges("|Y and >X").fillet(GROOVE_R_IN)

groove = outer.cut(inner)
# round the two inner corners at the closed end of the groove
groove = groove.edges(
    cq.selectors.BoxSelector((x_left - 0.1, -10, -in_top - 0.1), (x_left + 0.1, 10, in_top + 0.1))
).fillet(GROOVE_END_R)

result = plate.cut(groove)
